import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 72.0          # body width (X)
LB = 88.0         # main body length (Y), without hinge knuckles
H = 13.3          # body height (Z)
CH = 1.75         # chamfer on the top outline and on the side-face outline

# hinge knuckles at the two +Y corners
KW = 13.3         # knuckle width along X
KR = 3.35         # knuckle outer radius
KYC = LB + 4.0    # knuckle axis Y
KZC = 6.7         # knuckle axis Z
PIN_R = 2.2       # pin hole radius (cut after the chamfer)

# fixing ears, four on each long side
EAR_H = 5.2       # ear height
EAR_R = 3.3       # ear end radius
EAR_OFF = 3.2     # ear hole centre distance outside the wall
EAR_HOLE = 2.5    # ear hole diameter
EAR_HOLE_FIL = 0.4  # rounded entry of the ear hole
EAR_FIL = 0.5     # ear top edge rounding
EAR_ROOT = 0.5    # ear root fillet radius against the wall
EAR_Y0 = 10.8     # first ear position (from the front face)
EAR_PITCH = 21.3  # ear spacing
EAR_N = 4

# top dial recess
DISH_CY = LB / 2.0
DISH_R1 = 32.25   # outer shallow counterbore radius
DISH_D1 = 0.6
DISH_R2 = 30.15   # main recess radius
DISH_D2 = 2.25
SLOT_W = 8.0
SLOT_Y0 = 38.9    # slot end-centre positions
SLOT_Y1 = 70.2
SLOT_D = 1.0
SLOT_FIL = 0.4     # rounding of the slot rim
HOLE_D = SLOT_W - 0.02  # through hole at the slot end
HOLE_FIL = 0.3   # rounding of the hole rim under the ceiling

# underside pocket
RIM = 3.6         # wall thickness around the pocket at the bottom
POCKET_D = 9.0    # pocket ceiling height
POCKET_CH = 2.7   # chamfer between pocket walls and ceiling

# small vent hole in the -X wall
VENT_D = 2.2
VENT_Y = 64.0
VENT_Z = 2.8


# ---------------- helpers ----------------
def chamfer_edges(shape, edges, dist):
    return shape.chamfer(dist, None, list(edges))


def fillet_edges(shape, edges, rad):
    return shape.fillet(rad, list(edges))


def near(a, b, tol=1e-5):
    return abs(a - b) < tol


# ---------------- main body ----------------
body = cq.Workplane("XY").box(W, LB, H, centered=(True, False, False))

# knuckle side profile (drawn in the YZ plane, extruded along X)
P = (LB, H)
C = (KYC, KZC)
dx, dz = P[0] - C[0], P[1] - C[1]
d = math.hypot(dx, dz)
phi = math.atan2(dz, dx)
th = phi - math.acos(KR / d)                     # tangent point of the top slope
T = (C[0] + KR * math.cos(th), C[1] + KR * math.sin(th))
am = (th - math.pi / 2) / 2.0
M = (C[0] + KR * math.cos(am), C[1] + KR * math.sin(am))
zk = KZC - KR                                    # knuckle underside

prof = (
    cq.Workplane("YZ")
    .moveTo(LB - 2.0, zk)
    .lineTo(KYC, zk)
    .threePointArc(M, T)
    .lineTo(LB, H)
    .lineTo(LB - 2.0, H)
    .close()
)
knuckle = prof.extrude(KW)
body = (
    body.union(knuckle.translate((W / 2 - KW, 0, 0)))
    .union(knuckle.translate((-W / 2, 0, 0)))
)

# chamfer: every edge of the two side faces except the bottom one, plus the
# top edges of the front face and of the +Y face between the knuckles
sel = []
for e in body.val().Edges():
    a, b, c = e.startPoint(), e.endPoint(), e.Center()
    if a.z < 1e-6 and b.z < 1e-6:
        continue
    on_side = near(abs(a.x), W / 2) and near(abs(b.x), W / 2)
    top = near(a.z, H) and near(b.z, H)
    top_front = top and near(a.y, 0) and near(b.y, 0)
    top_gap = top and near(a.y, LB) and near(b.y, LB) and abs(c.x) < W / 2 - KW + 1e-6
    if on_side or top_front or top_gap:
        sel.append(e)
body = cq.Workplane("XY").add(chamfer_edges(body.val(), sel, CH))

# hinge pin hole through both knuckles
pin = (
    cq.Workplane("YZ")
    .workplane(offset=-W)
    .center(KYC, KZC)
    .circle(PIN_R)
    .extrude(2 * W)
)
body = body.cut(pin)

# ---------------- fixing ears ----------------
def ear_solid(y):
    """Lug on the +X wall at height 0..EAR_H, with root fillets to the wall."""
    xw = W / 2
    rf = EAR_ROOT
    r = EAR_R
    xc = xw + EAR_OFF
    s45 = math.sqrt(0.5)
    wp = (
        cq.Workplane("XY")
        .moveTo(xw - 1.0, y - r - rf)
        .lineTo(xw, y - r - rf)
        .threePointArc((xw + rf * (1 - s45), y - r - rf * (1 - s45)), (xw + rf, y - r))
        .lineTo(xc, y - r)
        .threePointArc((xc + r, y), (xc, y + r))
        .lineTo(xw + rf, y + r)
        .threePointArc((xw + rf * (1 - s45), y + r + rf * (1 - s45)), (xw, y + r + rf))
        .lineTo(xw - 1.0, y + r + rf)
        .close()
    )
    lug = wp.extrude(EAR_H)
    # round the exposed top edge
    tops = [
        e for e in lug.val().Edges()
        if near(e.startPoint().z, EAR_H) and near(e.endPoint().z, EAR_H)
        and e.Center().x > xw + 1e-3
    ]
    lug = fillet_edges(lug.val(), tops, EAR_FIL)
    # through hole with a rounded entry
    hole = cq.Solid.makeCylinder(EAR_HOLE / 2, EAR_H + 2, cq.Vector(xc, y, -1), cq.Vector(0, 0, 1))
    lug = lug.cut(hole)
    rim = [
        e for e in lug.Edges()
        if e.geomType() == "CIRCLE" and near(e.Center().z, EAR_H, 1e-3)
        and near(e.Center().x, xc, 1e-3) and near(e.Center().y, y, 1e-3)
    ]
    return fillet_edges(lug, rim, EAR_HOLE_FIL)


ear_pts = [EAR_Y0 + i * EAR_PITCH for i in range(EAR_N)]
ears = None
for y in ear_pts:
    e = ear_solid(y)
    for sh in (e, e.mirror("YZ")):
        ears = sh if ears is None else ears.fuse(sh)
body = body.union(cq.Workplane("XY").add(ears))

# ---------------- top dial recess ----------------
top = cq.Workplane("XY").workplane(offset=H)
body = body.cut(top.center(0, DISH_CY).circle(DISH_R1).extrude(-DISH_D1))
body = body.cut(top.center(0, DISH_CY).circle(DISH_R2).extrude(-(DISH_D1 + DISH_D2)))
zf = H - DISH_D1 - DISH_D2                       # dish floor
zs = zf - SLOT_D                                 # slot floor
slot = (
    cq.Workplane("XY")
    .workplane(offset=zs)
    .center(0, (SLOT_Y0 + SLOT_Y1) / 2)
    .slot2D(SLOT_Y1 - SLOT_Y0 + SLOT_W, SLOT_W, angle=90)
    .extrude(H - DISH_D1 - zs)
)
body = body.cut(slot)
# soften the slot rim on the dish floor
rim_edges = [
    e for e in body.val().Edges()
    if near(e.startPoint().z, zf) and near(e.endPoint().z, zf)
    and abs(e.Center().x) <= SLOT_W / 2 + 1e-3
    and SLOT_Y0 - SLOT_W / 2 - 1e-3 <= e.Center().y <= SLOT_Y1 + SLOT_W / 2
]
body = cq.Workplane("XY").add(fillet_edges(body.val(), rim_edges, SLOT_FIL))
# through hole under the slot end (continues the slot end wall downwards)
hole = cq.Workplane("XY").center(0, SLOT_Y1).circle(HOLE_D / 2).extrude(zs)
body = body.cut(hole)

# ---------------- underside pocket ----------------
pocket = (
    cq.Workplane("XY")
    .center(0, LB / 2)
    .rect(W - 2 * RIM, LB - 2 * RIM)
    .extrude(POCKET_D)
)
pocket = pocket.faces(">Z").edges().chamfer(POCKET_CH)
body = body.cut(pocket)
# round the lower rim of the through hole on the pocket ceiling
hole_rim = [
    e for e in body.val().Edges()
    if e.geomType() == "CIRCLE" and near(e.Center().z, POCKET_D, 1e-3)
    and abs(e.Center().x) < 1e-3 and near(e.Center().y, SLOT_Y1, 1e-3)
]
if HOLE_FIL > 0 and hole_rim:
    body = cq.Workplane("XY").add(fillet_edges(body.val(), hole_rim, HOLE_FIL))

# ---------------- small vent hole in the -X wall ----------------
vent = (
    cq.Workplane("YZ")
    .workplane(offset=-W / 2 - 1)
    .center(VENT_Y, VENT_Z)
    .circle(VENT_D / 2)
    .extrude(RIM + 2)
)
body = body.cut(vent)

result = body
